import math
import cadquery as cq
from OCP.BRepBuilderAPI import BRepBuilderAPI_NurbsConvert
from OCP.BRepIntCurveSurface import BRepIntCurveSurface_Inter
from OCP.gp import gp_Lin, gp_Pnt, gp_Dir

# =====================================================================
# Horseshoe shaped body: two front lobes (flat chamfered end faces) joined
# around the back, a raised crowned pad in the middle, a recessed saddle
# between the lobes carrying two pegs, and two stepped bosses on top.
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
LOBE_HW = 18.05        # half width of the lobe cross-section
LOBE_XC = 31.0         # centre line of the straight lobes (x)
Y_JOIN = -14.0         # straight lobes -> elliptic back
BACK_B = 28.55         # centre line ellipse semi-axis in y (back)
Y_SEC = -27.5          # back of the chamfer band (front of the swept body)
R_BOT = 11.0           # outer bottom round of the lobe section
R_SHOULDER = 6.0       # round between lobe wall and crown arch

# lobe section heights (outer wall top, crown peak, inner wall top)
# at the front, at the straight/elliptic join and at the back
SEC_FRONT = (26.5, 34.8, 23.0)
SEC_JOIN = (28.5, 36.8, 31.0)
SEC_BACK = (30.2, 38.6, 36.5)

# front chamfer band of the lobe faces
BAND = 4.9            # depth of the band at the lobe centre line
BAND_IN = 2.2
TOE_DEG = 5.5          # end faces turned so their outer edges lead
R_LOBE_IN_BOT = 11.0   # inner bottom corner of the lobe faces

# recessed saddle / neck between the lobes
NECK_Z_BACK = 30.9     # neck floor height at the pad front
NECK_Z_FRONT = 30.0    # neck floor height at the saddle front
SADDLE_HW = 13.4       # saddle half width behind the neck
NECK_HW_FRONT = 15.5   # neck half width at the saddle front
R_SADDLE_TOP = 7.0
R_SADDLE_BOT = 2.5

# central raised pad: egg shape in plan, cylindrical crown (axis along X)
PAD_R = 18.0
PAD_YC = 1.6
PAD_FRONT_Y = -13.5
PAD_FRONT_HW = 12.5
PAD_CYL_YC, PAD_CYL_ZC, PAD_CYL_R = 19.27, -24.44, 66.56
PAD_EDGE_R = 1.5

# pegs on the saddle front
PEG_X = 13.1
PEG_Z = 18.0
PEG_W = 13.0
PEG_H = 12.6
PEG_CH = 2.8            # outer corner round of the pegs
PEG_FRONT_Y = -34.1

# bosses on the lobe tops
BOSS_X = 28.2
BOSS_Y = -17.5
TEAR_R = 6.2           # front (big) round of the teardrop pad
TEAR_R2 = 3.8          # back (small) round of the teardrop pad
TEAR_LEN = 16.3        # overall length of the teardrop pad
TEAR_H = 2.0
TEAR_DRAFT = 30.0       # side draft of the teardrop pad
RING_R = 4.2
RING_H = 0.5
BOSS_R = 3.2
BOSS_H = 1.7

VIEW = {"azimuth": 45, "elevation": 26}

Y_FRONT = Y_SEC - BAND


# ---------------- lobe cross-section ----------------
def _circle3(p1, p2, p3):
    """centre and radius of the circle through three 2D points"""
    (x1, y1), (x2, y2), (x3, y3) = p1, p2, p3
    d = 2 * (x1 * (y2 - y3) + x2 * (y3 - y1) + x3 * (y1 - y2))
    ux = ((x1 ** 2 + y1 ** 2) * (y2 - y3) + (x2 ** 2 + y2 ** 2) * (y3 - y1) + (x3 ** 2 + y3 ** 2) * (y1 - y2)) / d
    uy = ((x1 ** 2 + y1 ** 2) * (x3 - x2) + (x2 ** 2 + y2 ** 2) * (x1 - x3) + (x3 ** 2 + y3 ** 2) * (x2 - x1)) / d
    return ux, uy, math.hypot(x1 - ux, y1 - uy)


def lobe_profile(P, n, v_out, v_p, v_in):
    """Closed lobe section wire. P: point on the centre line (z=0),
    n: outward horizontal unit vector; v_out / v_in: outer / inner wall
    top, v_p: crown peak (at the centre line)."""
    P = cq.Vector(P)
    n = cq.Vector(n)
    Z = cq.Vector(0, 0, 1)
    hw = LOBE_HW
    r = R_SHOULDER

    def pt(u, v):
        return P + n * u + Z * v

    cu, cv, ra = _circle3((hw, v_out), (0.0, v_p), (-hw, v_in))

    def shoulder(side):
        # fillet between the wall u = side*hw and the crown circle
        fu = side * (hw - r)
        fv = cv + math.sqrt((ra - r) ** 2 - (fu - cu) ** 2)
        L = math.hypot(fu - cu, fv - cv)
        tu, tv = cu + (fu - cu) / L * ra, cv + (fv - cv) / L * ra
        a0 = 0.0 if side > 0 else math.pi
        a1 = math.atan2(tv - fv, tu - fu)
        am = 0.5 * (a0 + a1)
        return (side * hw, fv), (fu + r * math.cos(am), fv + r * math.sin(am)), (tu, tv)

    (wo, mo, to) = shoulder(1)
    (wi, mi, ti) = shoulder(-1)
    am = -math.pi / 4
    e = [
        cq.Edge.makeLine(pt(-hw, 0), pt(hw - R_BOT, 0)),
        cq.Edge.makeThreePointArc(
            pt(hw - R_BOT, 0), pt(hw - R_BOT + R_BOT * math.cos(am), R_BOT + R_BOT * math.sin(am)), pt(hw, R_BOT)
        ),
        cq.Edge.makeLine(pt(hw, R_BOT), pt(*wo)),
        cq.Edge.makeThreePointArc(pt(*wo), pt(*mo), pt(*to)),
        cq.Edge.makeThreePointArc(pt(*to), pt(0, v_p), pt(*ti)),
        cq.Edge.makeThreePointArc(pt(*ti), pt(*mi), pt(*wi)),
        cq.Edge.makeLine(pt(*wi), pt(-hw, 0)),
    ]
    return cq.Wire.assembleEdges(e)


# ---------------- swept horseshoe body ----------------
path = cq.Wire.assembleEdges(
    [
        cq.Edge.makeLine(cq.Vector(-LOBE_XC, Y_SEC, 0), cq.Vector(-LOBE_XC, Y_JOIN, 0)),
        cq.Edge.makeEllipse(
            LOBE_XC, BACK_B, pnt=cq.Vector(0, Y_JOIN, 0), dir=cq.Vector(0, 0, -1),
            xdir=cq.Vector(-1, 0, 0), angle1=0, angle2=180,
        ),
        cq.Edge.makeLine(cq.Vector(LOBE_XC, Y_JOIN, 0), cq.Vector(LOBE_XC, Y_SEC, 0)),
    ]
)
sections = [
    lobe_profile((-LOBE_XC, Y_SEC, 0), (-1, 0, 0), *SEC_FRONT),
    lobe_profile((-LOBE_XC, Y_JOIN, 0), (-1, 0, 0), *SEC_JOIN),
    lobe_profile((0, Y_JOIN + BACK_B, 0), (0, 1, 0), *SEC_BACK),
    lobe_profile((LOBE_XC, Y_JOIN, 0), (1, 0, 0), *SEC_JOIN),
    lobe_profile((LOBE_XC, Y_SEC, 0), (1, 0, 0), *SEC_FRONT),
]
horseshoe = cq.Solid.sweep_multi(sections, path, True, False).fix()
body = cq.Workplane("XY").add(horseshoe)

# ---------------- saddle / neck filling the gap between the lobes ----------------
# plan: narrow at the pad front, flaring out over the lobe shoulders at the front
neck_slope = (NECK_Z_BACK - NECK_Z_FRONT) / (PAD_FRONT_Y - Y_SEC)
y_end = 5.0
saddle_plan = (
    cq.Workplane("XY")
    .polyline([(-NECK_HW_FRONT, Y_SEC), (NECK_HW_FRONT, Y_SEC), (SADDLE_HW, PAD_FRONT_Y),
               (SADDLE_HW, y_end), (-SADDLE_HW, y_end), (-SADDLE_HW, PAD_FRONT_Y)])
    .close()
    .extrude(50)
)
z_end = NECK_Z_BACK + (y_end - PAD_FRONT_Y) * neck_slope
saddle_side = (
    cq.Workplane("YZ", origin=(-30, 0, 0))
    .polyline([(Y_SEC - 1, -1), (y_end + 1, -1), (y_end + 1, z_end), (Y_SEC, NECK_Z_FRONT), (Y_SEC - 1, NECK_Z_FRONT)])
    .close()
    .extrude(60)
)
saddle = saddle_plan.intersect(saddle_side)
saddle = saddle.faces("<Y").edges("|X").edges("<Z").chamfer(R_SADDLE_BOT)
saddle = saddle.faces("<Y").edges("|X").edges(">Z").fillet(R_SADDLE_TOP)
body = body.union(saddle)

# ---------------- lobe end caps with chamfer band ----------------
def lobe_cap(sign):
    w = lobe_profile((sign * LOBE_XC, Y_SEC, 0), (sign, 0, 0), *SEC_FRONT)
    f = cq.Face.makeFromWires(w)
    vb = [v for v in f.Vertices() if abs(abs(v.X) - (LOBE_XC - LOBE_HW)) < 1e-6 and v.Z < 1e-6]
    f = f.fillet2D(R_LOBE_IN_BOT, vb)
    w0 = f.outerWire()
    w1 = w0.offset2D(-BAND_IN, "arc")[0]
    w1 = cq.Shape.cast(BRepBuilderAPI_NurbsConvert(w1.wrapped, True).Shape())
    w1 = w1.translate(cq.Vector(0, -BAND, 0))
    # toe the end face: outer edge forward, inner edge back
    w1 = w1.rotate(cq.Vector(sign * LOBE_XC, Y_FRONT, 0), cq.Vector(sign * LOBE_XC, Y_FRONT, 1), -sign * TOE_DEG)
    return cq.Solid.makeLoft([w0, w1], True)


body = body.union(cq.Workplane().add(lobe_cap(-1))).union(cq.Workplane().add(lobe_cap(1)))

# ---------------- central crowned pad ----------------
# flanks run from the front corners tangent into the round back
_dx, _dy = PAD_FRONT_HW, PAD_FRONT_Y - PAD_YC
_d = math.hypot(_dx, _dy)
_ang = math.atan2(_dy, _dx) + math.acos(PAD_R / _d)
_tx, _ty = PAD_R * math.cos(_ang), PAD_YC + PAD_R * math.sin(_ang)
egg = (
    cq.Workplane("XY")
    .moveTo(-PAD_FRONT_HW, PAD_FRONT_Y)
    .lineTo(PAD_FRONT_HW, PAD_FRONT_Y)
    .lineTo(_tx, _ty)
    .threePointArc((0, PAD_YC + PAD_R), (-_tx, _ty))
    .close()
)
egg_prism = egg.extrude(60).translate((0, 0, 5))
pad_cyl = cq.Workplane("YZ").center(PAD_CYL_YC, PAD_CYL_ZC).circle(PAD_CYL_R).extrude(60, both=True)
pad_solid = egg_prism.intersect(pad_cyl)
pad_solid = pad_solid.faces(">Z").edges().fillet(PAD_EDGE_R)
body = body.cut(egg_prism).union(pad_solid)


# ---------------- pegs ----------------
def peg(sign):
    xo = -PEG_X - PEG_W / 2          # outer x of the left peg
    r = PEG_H / 2
    xc = xo + (PEG_W - r)            # centre of the inner round
    zc = PEG_Z
    c = PEG_CH
    k = math.sqrt(0.5)
    y0 = Y_SEC + 3
    w = (
        cq.Workplane("XZ", origin=(0, y0, 0))
        .moveTo(xc, zc - r)
        .threePointArc((xc + r, zc), (xc, zc + r))
        .lineTo(xo + c, zc + r)
        .threePointArc((xo + c - c * k, zc + r - c + c * k), (xo, zc + r - c))
        .lineTo(xo, zc - r + c)
        .threePointArc((xo + c - c * k, zc - r + c - c * k), (xo + c, zc - r))
        .close()
        .extrude(y0 - PEG_FRONT_Y)
    )
    w = w.faces("<Y").edges().fillet(0.8)
    if sign > 0:
        w = w.mirror("YZ")
    return w


body = body.union(peg(-1)).union(peg(1))


# ---------------- bosses on the lobe tops ----------------
def top_z(shape, x, y):
    """Highest point of the body surface above (x, y)."""
    inter = BRepIntCurveSurface_Inter()
    inter.Init(shape.wrapped, gp_Lin(gp_Pnt(x, y, 100.0), gp_Dir(0, 0, -1)), 1e-6)
    zs = []
    while inter.More():
        zs.append(inter.Pnt().Z())
        inter.Next()
    return max(zs)


def boss(sign):
    x = sign * BOSS_X
    h = 1.5
    z0 = top_z(horseshoe, x, BOSS_Y)
    zx = top_z(horseshoe, x + h, BOSS_Y)
    zy = top_z(horseshoe, x, BOSS_Y + h)
    nrm = cq.Vector(-(zx - z0) / h, -(zy - z0) / h, 1).normalized()
    xd = cq.Vector(0, 1, 0).cross(nrm).normalized()     # local x, local y ~ +Y
    pl = cq.Plane(origin=(x, BOSS_Y, z0), xDir=xd, normal=nrm)
    L = TEAR_LEN - TEAR_R - TEAR_R2                     # distance between the rounds
    a = math.asin((TEAR_R - TEAR_R2) / L)
    ca, sa = math.cos(a), math.sin(a)
    sink = 1.0                                          # start below the surface
    grow = sink * math.tan(math.radians(TEAR_DRAFT))
    r1, r2 = TEAR_R + grow, TEAR_R2 + grow
    tear = (
        cq.Workplane(pl)
        .workplane(offset=-sink)
        .moveTo(-r1 * ca, r1 * sa)
        .threePointArc((0, -r1), (r1 * ca, r1 * sa))
        .lineTo(r2 * ca, L + r2 * sa)
        .threePointArc((0, L + r2), (-r2 * ca, L + r2 * sa))
        .close()
        .extrude(sink + TEAR_H, taper=TEAR_DRAFT)
    )
    stud = (
        cq.Workplane(pl)
        .workplane(offset=TEAR_H - 0.5)
        .circle(RING_R)
        .extrude(RING_H + 0.5)
        .faces(">Z")
        .workplane()
        .circle(BOSS_R)
        .extrude(BOSS_H)
    )
    return tear.union(stud)


body = body.union(boss(-1)).union(boss(1))

result = body
